import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
LX = 72.5          # outer length along X
LY = 75.0          # outer length along Y
H = 12.2           # overall height
R_L = 12.0         # outer plan radius of the two -X corners
R_R = 9.3          # outer plan radius of the two +X corners
T = 3.1            # wall thickness
FLOOR = 3.1        # floor thickness
EDGE_C = 0.95      # chamfer of the outer top / bottom edges on the straight sides
BEV_H = 1.3        # shallow bevel all round the underside (horizontal width)
BEV_V = 0.25       # shallow bevel all round the underside (height)

BOSS_H = 3.5       # height of the half-disc bosses above the floor

PITCH = 2.54
PIN_D = 1.1


def rounded_rect(w, h, r_bl, r_br, r_tr, r_tl):
    """Closed plan outline (centred) with an individual radius per corner."""
    x0, x1 = -w / 2, w / 2
    y0, y1 = -h / 2, h / 2
    k = 1 - math.sqrt(0.5)
    wp = (cq.Workplane("XY")
          .moveTo(x0 + r_bl, y0)
          .lineTo(x1 - r_br, y0)
          .threePointArc((x1 - r_br * k, y0 + r_br * k), (x1, y0 + r_br))
          .lineTo(x1, y1 - r_tr)
          .threePointArc((x1 - r_tr * k, y1 - r_tr * k), (x1 - r_tr, y1))
          .lineTo(x0 + r_tl, y1)
          .threePointArc((x0 + r_tl * k, y1 - r_tl * k), (x0, y1 - r_tl))
          .lineTo(x0, y0 + r_bl)
          .threePointArc((x0 + r_bl * k, y0 + r_bl * k), (x0 + r_bl, y0))
          .close())
    return wp


# ---------------- outer body ----------------
body = rounded_rect(LX, LY, R_L, R_R, R_R, R_L).extrude(H)
body = body.faces("<Z").edges().chamfer(BEV_V, BEV_H)

# sharp box with chamfered horizontal edges: intersecting it with the rounded
# body gives edge chamfers on the straight sides that fade out around the corners
rbox = (cq.Workplane("XY").box(LX, LY, H, centered=(True, True, False))
        .edges("not |Z").chamfer(EDGE_C))
body = body.intersect(rbox)

# ---------------- pocket ----------------
IX, IY = LX - 2 * T, LY - 2 * T
inner = rounded_rect(IX, IY, R_L - T, R_R - T, R_R - T, R_L - T).extrude(H)
body = body.cut(inner.translate((0, 0, FLOOR)))

# ---------------- half-disc bosses against the walls ----------------
xi = IX / 2
yi = IY / 2


def boss(cx, cy, r):
    return (cq.Workplane("XY").workplane(offset=FLOOR - 0.01)
            .center(cx, cy).circle(r).extrude(BOSS_H + 0.01))


bosses = (boss(-19.3, yi, 10.6)
          .union(boss(-xi, 0.0, 6.15))
          .union(boss(xi, 0.1, 6.1))
          .union(boss(1.3, -yi, 6.15)))
bosses = bosses.intersect(inner)
body = body.union(bosses)

# ---------------- scallops in the -X wall ----------------
SC_R = 9.3
SC_DEPTH = 3.1
for yc in (17.1, -9.25):
    cyl = (cq.Workplane("YZ").workplane(offset=-LX / 2 - 1)
           .center(yc, H - SC_DEPTH + SC_R).circle(SC_R).extrude(T + 2))
    body = body.cut(cyl)

# U-notch next to the (-X,-Y) corner
NOTCH_Y = -27.25
NOTCH_W = 6.5
NOTCH_D = 5.2
nr = NOTCH_W / 2
notch_wp = cq.Workplane("YZ").workplane(offset=-LX / 2 - 1)
zc = H - NOTCH_D + nr
notch = (notch_wp.center(NOTCH_Y, zc).rect(NOTCH_W, H - zc + 1, centered=(True, False))
         .extrude(T + 4))
notch = notch.union(cq.Workplane("YZ").workplane(offset=-LX / 2 - 1)
                    .center(NOTCH_Y, zc).circle(nr).extrude(T + 4))
body = body.cut(notch)

# USB notch in the +Y wall: chamfered shoulders, then steep, then sloped to a flat bottom
USB_X = 10.1
USB_W_TOP = 13.0
USB_W_BOT = 8.8
USB_D = 3.3
hw_t = USB_W_TOP / 2
hw_b = USB_W_BOT / 2
half = [(hw_t, H), (hw_t - 0.9, H - 0.9), (hw_t - 1.3, H - 2.1), (hw_b, H - USB_D)]
prof = ([(USB_X - dx, z) for dx, z in half]
        + [(USB_X + dx, z) for dx, z in reversed(half)]
        + [(USB_X + hw_t + 2, H + 2), (USB_X - hw_t - 2, H + 2)])
usb = (cq.Workplane("XZ").workplane(offset=-(LY / 2 + 1))
       .polyline(prof).close()
       .extrude(T + 2))
body = body.cut(usb)

# ---------------- floor holes (Pico style footprint + extras) ----------------
colA = 1.2
colB = colA + 7 * PITCH
y0 = 30.6
pts = []
for i in range(20):
    pts.append((colA, y0 - i * PITCH))
    pts.append((colB, y0 - i * PITCH))
xc = (colA + colB) / 2
for k in (-1, 0, 1):
    pts.append((xc + k * PITCH, y0 - 19 * PITCH))
for i in range(4):
    pts.append((-23.0, 7.64 - i * PITCH))
pts += [(-16.6, -11.4), (-9.0, -11.4)]
pts += [(-26.2, -25.4), (-26.2, -28.0)]


def holes(points, d):
    w = cq.Workplane("XY").workplane(offset=-1)
    return w.pushPoints(points).circle(d / 2).extrude(FLOOR + 2)


body = body.cut(holes(pts, PIN_D))
body = body.cut(holes([(7.4, 30.5), (12.9, 30.5)], 1.7))
body = body.cut(holes([(7.7, 27.4), (12.6, 27.4)], 1.4))

result = body
